import math
import cadquery as cq

# =====================================================================
#  Rear-right ("RR") corner hopper piece: two walls at 90 deg with a
#  chamfered corner, vertical upper parts and inward sloping lower parts,
#  joggled end flanges, inner ledges, bottom flange and a rear bracket.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 200.0        # length of back wall (X); outer face of side wall at X=W
D = 154.0        # length of side wall (Y); outer face of back wall at Y=D
H = 120.0        # height at the back
H_FRONT = 111.5  # height of the side wall top at its front end (Y=0)
T = 6.0          # wall thickness

ZS = 51.0        # side wall bend height
KS = 0.667       # side wall lower slope (run / rise)
ZB = 36.0        # back wall bend height
KB = 0.667       # back wall lower slope (run / rise)
C_TOP = 10.7     # corner chamfer at the top (X+Y offset)
C_RATE = 0.38    # corner chamfer growth per mm of depth


FL_W = 16.0      # width of the back wall end flange
SFL_W = 17.5     # width of the side wall end flange
SJOG = 3.5       # rebate of the side wall flange (outer side)
SFL_T = T - SJOG # side flange thickness (flush with the inner face)
BFL_T = T + 1.0  # back wall flange thickness (flush outside)
BF_Z0 = 30.0     # bottom of the back wall flange

TOP_CH = 0.6     # chamfer on the inner top edge
LEDGE_Z = 88.3   # top of the inner ledges
LEDGE_D = 8.3    # ledge depth
LEDGE_F = 5.7    # ledge front face height
LEDGE_H = 23.3   # total ledge height (underside meets the wall)
LEDGE_X0 = 16.6  # start of the back ledge
SLEDGE_Y0, SLEDGE_L = 19.0, 43.0   # short ledge on the side wall
SLEDGE_D, SLEDGE_F, SLEDGE_H = 5.8, 1.5, 11.5   # its depth, front face, height

BASE_T = 4.5     # bottom flange thickness
BASE_IN = 1.3    # bottom flange inward projection
GUSSET = (16.0, 31.0)   # corner gusset of the bottom flange (dx, dy)

TRIM_C = 171.0   # back slope trimmed where X + Y < TRIM_C (screw access)

BR_Y1 = D + 10.5   # rear face of the rear bracket
BR_Z1 = ZB + 0.7   # top of the rear bracket
BR_C = 176.0       # chamfer plane X + Y = BR_C of the bracket / web face
BR_CH = 5.0        # bracket edge chamfer
REL_X0, REL_K = 2.0, 0.646   # inclined relief X <= REL_X0 + REL_K*Z
BR_GX, BR_GW, BR_GD = 4.5, 1.8, 1.5   # groove in the bracket rear face (x, width, depth)

BIG = 2000.0


# ---------------- helpers ----------------
def unit(v):
    l = math.sqrt(sum(c * c for c in v))
    return tuple(c / l for c in v)


def cross(a, b):
    return (a[1] * b[2] - a[2] * b[1], a[2] * b[0] - a[0] * b[2], a[0] * b[1] - a[1] * b[0])


def neg(v):
    return tuple(-c for c in v)


def halfspace(p, n):
    """Solid region {x : (x-p).n <= 0} (bounded by a big box)."""
    n = unit(n)
    ref = (0, 0, 1) if abs(n[2]) < 0.9 else (1, 0, 0)
    pl = cq.Plane(origin=p, xDir=cross(ref, n), normal=n)
    return cq.Workplane(pl).rect(BIG, BIG).extrude(-BIG)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def offset_pt(p, n, d):
    u = unit(n)
    return (p[0] - u[0] * d, p[1] - u[1] * d, p[2] - u[2] * d)


# wall planes (point, outward normal)
N_SIDE, P_SIDE = (1.0, 0.0, 0.0), (W, 0.0, 0.0)
N_SSLOPE, P_SSLOPE = (1.0, 0.0, -KS), (W, 0.0, ZS)
N_BACK, P_BACK = (0.0, 1.0, 0.0), (0.0, D, 0.0)
N_BSLOPE, P_BSLOPE = (0.0, 1.0, -KB), (0.0, D, ZB)
N_CORNER, P_CORNER = (1.0, 1.0, -C_RATE), (W, D - C_TOP, H)
N_TOP, P_TOP = (0.0, -(H - H_FRONT) / D, 1.0), (0.0, 0.0, H_FRONT)

WALL_PLANES = [(P_SIDE, N_SIDE), (P_SSLOPE, N_SSLOPE), (P_BACK, N_BACK),
               (P_BSLOPE, N_BSLOPE), (P_CORNER, N_CORNER)]


def envelope(offset, top=True, bounded=True):
    """Intersection of the wall half spaces moved inwards by `offset`."""
    if bounded:
        s = box(0, W, 0, D, 0, H + 5)
    else:
        s = box(-300, W + 300, -300, D + 300, -300, H + 300)
    for p, n in WALL_PLANES:
        s = s.intersect(halfspace(offset_pt(p, n, offset), n))
    if top:
        s = s.intersect(halfspace(P_TOP, N_TOP))
    return s


def shell_between(o0, o1, top=True):
    """Wall material between the inward offsets o0 < o1."""
    a = envelope(o0, top=top, bounded=True) if o0 == 0 else \
        envelope(o0, top=top, bounded=False).intersect(box(0, W, 0, D, 0, H + 5))
    return a.cut(envelope(o1, top=False, bounded=False))


# ---------------- main hopper walls ----------------
outer = envelope(0.0)
walls = shell_between(0.0, T)


# small 45 deg chamfer along the inner top edge of the walls
t_up = unit(N_TOP)
VERT_WALLS = [(P_SIDE, N_SIDE), (P_BACK, N_BACK), (P_CORNER, N_CORNER)]
for i, (pi, ni) in enumerate(VERT_WALLS):
    nu = unit(ni)
    q = offset_pt(pi, ni, T)                      # point on the inner face
    m = tuple(nu[k] - t_up[k] for k in range(3))  # (n - t)
    # u + v < TOP_CH  <=>  p.(n - t) < TOP_CH + q.n - top.t
    c0 = TOP_CH + sum(q[k] * nu[k] for k in range(3)) - sum(P_TOP[k] * t_up[k] for k in range(3))
    mm = math.sqrt(sum(c * c for c in m))
    ref_pt = tuple(m[k] / mm * (c0 / mm) for k in range(3))
    region = halfspace(ref_pt, m)
    for j, (pj, nj) in enumerate(WALL_PLANES):
        if pj == pi and nj == ni:
            continue
        region = region.intersect(halfspace(offset_pt(pj, nj, T), nj))
    walls = walls.cut(region.intersect(box(FL_W, W + 5, -5, D + 5, H - 30, H + 10))
                      .intersect(box(-5, W + 5, SFL_W, D + 5, H - 30, H + 10)))

# ---------------- joggled side wall flange (front end) ----------------
fl_zone = box(W - 80, W + 1, -1, SFL_W, -1, H + 10)
side_fl = shell_between(SJOG, SJOG + SFL_T).intersect(fl_zone)
step = shell_between(0.0, T).intersect(box(W - 80, W + 1, SFL_W - 1.0, SFL_W, -1, H + 10))
walls = walls.cut(fl_zone).union(side_fl).union(step)

# ---------------- back wall flange (-X end) ----------------
back_fl = (box(0, FL_W, D - BFL_T, D, BF_Z0, H + 5)
           .intersect(halfspace(P_TOP, N_TOP)))
walls = walls.cut(box(-1, FL_W, D - 60, D + 1, BF_Z0, H + 10)).union(back_fl)

# ---------------- -X end, lower part ----------------
# the back slope is trimmed by a vertical 45 deg plane (screw access)
walls = walls.cut(box(-1, 80, D - 60, D + 1, -1, ZB + 0.01)
                  .intersect(halfspace((TRIM_C, 0.0, 0.0), (1.0, 1.0, 0.0))))

# rear bracket profile (YZ) with chamfered rear edges
br_prof = (cq.Workplane("YZ")
           .polyline([(90.0, 0), (BR_Y1 - BR_CH, 0), (BR_Y1, BR_CH),
                      (BR_Y1, BR_Z1 - BR_CH), (BR_Y1 - BR_CH, BR_Z1), (90.0, BR_Z1)])
           .close().extrude(60.0))

# end support: end web in the wall plane + bracket behind it, relieved by an
# inclined (overhanging) plane
support = (box(0, 60, D - T, D + 0.01, 0, BF_Z0 + 0.5)
           .union(box(0, 60, D, BR_Y1, 0, BR_Z1))
           .intersect(br_prof)
           .intersect(halfspace((REL_X0, 0.0, 0.0), (1.0, 0.0, -REL_K)))
           .intersect(halfspace((BR_C, 0.0, 0.0), (1.0, 1.0, 0.0))))
walls = walls.union(support)
# vertical groove in the rear face of the bracket
walls = walls.cut(box(BR_GX, BR_GX + BR_GW, BR_Y1 - BR_GD, BR_Y1 + 1, -1, BR_Z1 + 1))

# web closing the trimmed end of the slope, lying in the 45 deg trim plane
P_BSLOPE_IN = offset_pt(P_BSLOPE, N_BSLOPE, T)
web = (box(0, 60, 100, BR_Y1, 0, BR_Z1)
       .intersect(br_prof)
       .intersect(halfspace((TRIM_C, 0.0, 0.0), (-1.0, -1.0, 0.0)))
       .intersect(halfspace((BR_C, 0.0, 0.0), (1.0, 1.0, 0.0)))
       .intersect(halfspace(P_BSLOPE_IN, neg(N_BSLOPE))))
walls = walls.union(web)


# ---------------- ledges on the inner faces ----------------
def ledge_solid(plane_name, wall_coord, length, offset_vec, depth, front, height):
    """Short ledge: flat top, short front face and smooth underside running
    back into the wall.  u = distance from the wall face."""
    z0 = LEDGE_Z - height
    z1 = LEDGE_Z - front

    def c(u):
        return wall_coord - u
    wp = (cq.Workplane(plane_name)
          .moveTo(c(-0.6), LEDGE_Z).lineTo(c(depth), LEDGE_Z)
          .lineTo(c(depth), z1)
          .spline([(c(depth * 0.42), (z1 + z0) / 2.0 - 0.5), (c(-0.3), z0)],
                  tangents=[(0.0, -1.0), (0.25, -1.0)], includeCurrent=True)
          .lineTo(c(-0.6), z0).close())
    return wp.extrude(length).translate(offset_vec)


# back wall ledge: its S-shaped underside forms one smooth face that runs
# all the way down to the bend of the back wall
yb = D - T
ZB_IN = ZB + T * math.tan(0.5 * math.atan(KB))      # inner bend height
z_end = ZB_IN - 1.5
u_end = KB * (ZB_IN - z_end)
bl = (cq.Workplane("YZ")
      .moveTo(yb + 0.6, LEDGE_Z).lineTo(yb - LEDGE_D, LEDGE_Z)
      .spline([(yb - LEDGE_D + 0.6, LEDGE_Z - LEDGE_F),
               (yb - LEDGE_D * 0.45, LEDGE_Z - 0.55 * LEDGE_H),
               (yb - 0.7, LEDGE_Z - LEDGE_H),
               (yb - 0.35, 0.5 * (LEDGE_Z - LEDGE_H + z_end)),
               (yb - u_end, z_end)],
              tangents=[(0.0, -1.0), (0.0, -1.0)], includeCurrent=True)
      .lineTo(yb + 0.6, z_end).close())
back_ledge = bl.extrude(W).translate((LEDGE_X0, 0, 0))
back_ledge = back_ledge.intersect(envelope(T - 0.6, top=False, bounded=False))
for xh in (19.7, 78.0, 117.0, 173.5):
    back_ledge = back_ledge.cut(
        cq.Workplane("XY").circle(2.2).extrude(5)
        .translate((xh, yb - 4.3, LEDGE_Z - 3.5)))
walls = walls.union(back_ledge)

xs = W - T
side_ledge = ledge_solid("XZ", xs, -SLEDGE_L, (0, SLEDGE_Y0, 0), SLEDGE_D, SLEDGE_F, SLEDGE_H)
walls = walls.union(side_ledge)

# ---------------- bottom flange / base plate ----------------
YB_IN = D - KB * ZB - T * math.sqrt(1 + KB * KB) - BASE_IN   # inner edge, back
XB_IN = W - KS * ZS - T * math.sqrt(1 + KS * KS) - BASE_IN   # inner edge, side
base_pts = [(-1, YB_IN), (XB_IN - GUSSET[0], YB_IN), (XB_IN, YB_IN - GUSSET[1]),
            (XB_IN, -1), (W, -1), (W, D + 20), (-1, D + 20)]
base = cq.Workplane("XY").polyline(base_pts).close().extrude(BASE_T)
base = base.intersect(outer.union(
    box(0, 60, D - 60, BR_Y1, 0, BASE_T).intersect(br_prof)
    .intersect(halfspace((BR_C, 0.0, 0.0), (1.0, 1.0, 0.0)))))
base = base.cut(box(W - 80, W + 1, -1, SFL_W - 1.0, -1, BASE_T + 1)
                .cut(envelope(SJOG, top=False, bounded=False)))
walls = walls.union(base)

# ear with a hole on the front edge of the base plate at the -X end
EAR_X, EAR_Y, EAR_R = 21.2, YB_IN - 2.2, 5.2
ear = cq.Workplane("XY").circle(EAR_R).extrude(BASE_T).translate((EAR_X, EAR_Y, 0))
walls = walls.union(ear)
for (hx, hy, r) in ((EAR_X, EAR_Y, 2.7), (24.9, 136.1, 2.2),
                    (XB_IN - 4.8, YB_IN - 4.9, 2.2)):
    walls = walls.cut(cq.Workplane("XY").circle(r).extrude(BASE_T + 2)
                      .translate((hx, hy, -1)))

# ---------------- holes ----------------
su = unit(N_SSLOPE)
bu = unit(N_BSLOPE)

# side flange holes (through X), two in the vertical part, two in the sloped part
for zh in (105.8, 60.8):
    walls = walls.cut(cq.Workplane("YZ").circle(2.0).extrude(30)
                      .translate((W - 20, 8.5, zh)))
for zh in (40.0, 11.5):
    walls = walls.cut(cq.Workplane("YZ").circle(2.0).extrude(60)
                      .translate((W - 60, 8.5, zh)))

# back flange holes (blind, drilled from the inside along Y)
for zh in (110.7, 46.6):
    walls = walls.cut(cq.Workplane("XZ").circle(2.1).extrude(-(BFL_T - 1.5 + 10))
                      .translate((8.2, D - BFL_T - 10, zh)))

# small blind pockets (pairs) on the inner faces of the slopes
TB = T * math.sqrt(1 + KB * KB)
TS = T * math.sqrt(1 + KS * KS)
for xh in (45.4, 96.4, 146.1):
    for zh in (30.6, 25.5):
        yc = D - KB * (ZB - zh) - TB
        pl = cq.Plane(origin=(xh, yc - 2.0 * bu[1], zh - 2.0 * bu[2]), xDir=(1, 0, 0), normal=bu)
        walls = walls.cut(cq.Workplane(pl).circle(1.1).extrude(3.5))
for yh in (97.2, 47.2):
    for zh in (23.8, 19.4):
        xc = W - KS * (ZS - zh) - TS
        pl = cq.Plane(origin=(xc - 2.0 * su[0], yh, zh - 2.0 * su[2]), xDir=(0, 1, 0), normal=su)
        walls = walls.cut(cq.Workplane(pl).circle(1.1).extrude(3.5))

# ---------------- "RR" marking engraved in the side slope ----------------
TXT_Y, TXT_Z, TXT_SIZE, TXT_DEPTH = 70.5, 24.5, 25.0, 0.6
try:
    n_in = neg(su)                                   # inner slope normal
    x_txt = W - TS - KS * (ZS - TXT_Z)
    tpl = cq.Plane(origin=(x_txt, TXT_Y, TXT_Z), xDir=(0.0, -1.0, 0.0), normal=n_in)
    txt = cq.Workplane(tpl).text("RR", TXT_SIZE, -TXT_DEPTH, combine=False)
    engraved = walls.cut(txt)
    if engraved.val().isValid():
        walls = engraved
except Exception:
    pass

result = walls
